import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HOLE_PITCH_Z = 100.0     # vertical distance between mounting holes
HOLE_PITCH_X = 50.0      # horizontal distance between mounting holes / lug centres
BAR_W = 20.0             # width of the two vertical lugs (end radius = BAR_W/2)
HUB_D = 75.0             # outer diameter of the central ring
BORE_D = 50.0            # central bore diameter
MOUNT_D = 8.8            # mounting (through) hole diameter
CBORE_D = 15.0           # counterbore diameter (on the +Y / back face)
CBORE_DEPTH = 6.2        # counterbore depth
THK = 8.7                # plate thickness (along Y)

BAR_LEN = HOLE_PITCH_Z + BAR_W   # overall length of each lug

# plate lies in the XZ plane, thickness along Y (centred on y=0)
# Workplane "XZ" has its normal along -Y, so start at +THK/2 and extrude THK
wp = cq.Workplane("XZ", origin=(0, THK / 2.0, 0))

bars = (
    wp.pushPoints([(-HOLE_PITCH_X / 2.0, 0), (HOLE_PITCH_X / 2.0, 0)])
    .slot2D(BAR_LEN, BAR_W, angle=90)
    .extrude(THK)
)
hub = wp.circle(HUB_D / 2.0).extrude(THK)
body = bars.union(hub)

# central bore
body = body.cut(
    cq.Workplane("XZ", origin=(0, THK, 0)).circle(BORE_D / 2.0).extrude(THK * 2)
)

# mounting holes with counterbores from the back (+Y) face
pts = [(sx * HOLE_PITCH_X / 2.0, sz * HOLE_PITCH_Z / 2.0)
       for sx in (-1, 1) for sz in (-1, 1)]
thru = cq.Workplane("XZ", origin=(0, THK, 0)).pushPoints(pts).circle(MOUNT_D / 2.0).extrude(THK * 2)
cbore = (
    cq.Workplane("XZ", origin=(0, THK / 2.0 + 1.0, 0))
    .pushPoints(pts)
    .circle(CBORE_D / 2.0)
    .extrude(CBORE_DEPTH + 1.0)
)
body = body.cut(thru).cut(cbore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
